import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Driving dimensions (mm)
# ---------------------------------------------------------------------------
# Long flat bar (lies diagonally in XY at 45 deg, flange end at -X/+Y,
# eye end at +X/-Y). Local frame: a = along bar, b = across bar, z = up.
BAR_W = 47.0          # bar width
BAR_T = 9.5           # bar thickness
BAR_TOP = 60.0        # bar top height above floor
HALF_LEN = 301.0      # centre -> outer end face

BLOCK_W = 49.0        # end blocks (slightly wider than the bar)
FL_BLOCK_L = 53.0     # flange-end block length
EYE_BLOCK_L = 31.0    # eye-end block length
BLOCK_STEP = 0.2      # end blocks stand this much proud of the bar top

# eye plate at +a end
EYE_T = 20.0          # plate thickness along bar
EYE_W = 48.0          # plate width
EYE_R = EYE_W / 2.0   # rounded bottom radius
EYE_ZC = 26.0         # hole centre height
EYE_HOLE_D = 23.0
EYE_CB_D = 36.0       # relief bore from the inner side
EYE_CB_DEPTH = 15.0

# 2-bolt flange bearing housing at -a end
FL_T = 22.5           # flange thickness
FL_TOP = 54.0         # flange top height
FL_TOP_HW = 24.4      # half width of flange top edge
FL_ZC = 26.0          # bore / bolt centre height
EAR_C = 30.0          # bolt centre distance from middle
EAR_R = 10.5          # ear radius
TIP_R = 12.0          # bottom tip radius
TIP_ZC = 13.0         # bottom tip centre height
BORE_D = 20.0         # through bore on the outer side
RECESS_D = 44.0       # bearing seat recess on the inner face
RECESS_DEPTH = 13.0
BOLT_D = 8.0
NUT_AF = 10.0         # hex nut pocket across flats
NUT_T = 2.5           # hex nut pocket depth

# vertical rod through the middle of the bar
ROD_D = 13.0
ROD_H = 336.0         # top height
ROD_Z0 = 1.5          # bottom height

# four standoff tiles
TILE = 29.4
TILE_GAP = 1.0
TILE_T = 7.0
PIN_D = 17.0
PIN_TOP = 40.0
PIN_HOLE_D = 6.5
PIN_HOLE_DEPTH = 24.0
PIN_CH = 1.0          # chamfer on the pin top
TILE_R = 1.5          # tile corner radius
PIN_OFF = 5.4         # pin offset from tile centre (+X, -Y)
PAD_X = -122.0        # centre of the 2x2 group
PAD_Y = -108.0

BAR_ANGLE = -45.0     # rotation of the local bar frame about Z


# ---------------------------------------------------------------------------
# helpers
# ---------------------------------------------------------------------------
def box(a0, a1, b0, b1, z0, z1):
    return (cq.Workplane("XY")
            .box(a1 - a0, b1 - b0, z1 - z0, centered=False)
            .translate((a0, b0, z0)))


def cyl_a(a0, length, b, z, r, seam_down=False):
    """Cylinder along the local bar axis (+a) centred at (b, z)."""
    c = cq.Solid.makeCylinder(r, length, cq.Vector(a0, b, z), cq.Vector(1, 0, 0))
    if seam_down:      # turn the seam line to the underside of the bore
        c = c.rotate(cq.Vector(a0, b, z), cq.Vector(a0 + 1, b, z), 180)
    return cq.Workplane("XY").add(c)


def hull_profile(wp, circles):
    """Closed convex outline wrapped around circles listed CCW as (x, y, r);
    r = 0 gives a sharp corner. Straight tangents joined by arcs."""
    n = len(circles)
    segs = []
    for i in range(n):
        x1, y1, r1 = circles[i]
        x2, y2, r2 = circles[(i + 1) % n]
        dx, dy = x2 - x1, y2 - y1
        L = math.hypot(dx, dy)
        ux, uy = dx / L, dy / L
        px, py = uy, -ux                  # right-hand normal = outside for CCW
        al = (r1 - r2) / L
        be = math.sqrt(max(0.0, 1 - al * al))
        nx, ny = al * ux + be * px, al * uy + be * py
        segs.append(((x1 + r1 * nx, y1 + r1 * ny), (x2 + r2 * nx, y2 + r2 * ny), (nx, ny)))
    wp = wp.moveTo(*segs[0][0])
    for i in range(n):
        _, p1, n1 = segs[i]
        wp = wp.lineTo(*p1)
        cx, cy, r = circles[(i + 1) % n]
        q0, _, n2 = segs[(i + 1) % n]
        if r > 1e-9:
            mx, my = n1[0] + n2[0], n1[1] + n2[1]
            ml = math.hypot(mx, my)
            wp = wp.threePointArc((cx + r * mx / ml, cy + r * my / ml), q0)
    return wp.close()


# ---------------------------------------------------------------------------
# bar body (built in the local a/b/z frame)
# ---------------------------------------------------------------------------
z_bot = BAR_TOP - BAR_T
a_fl_out = -HALF_LEN
a_eye_out = HALF_LEN
a_eye_in = a_eye_out - EYE_T
a_eyeblk_in = a_eye_in - EYE_BLOCK_L
a_flblk_in = a_fl_out + FL_BLOCK_L

bar = box(a_flblk_in, a_eyeblk_in, -BAR_W / 2, BAR_W / 2, z_bot, BAR_TOP)
blk_top = BAR_TOP + BLOCK_STEP
fl_block = box(a_fl_out, a_flblk_in, -BLOCK_W / 2, BLOCK_W / 2, z_bot, blk_top)
eye_block = box(a_eyeblk_in, a_eye_in, -BLOCK_W / 2, BLOCK_W / 2, z_bot, blk_top)

# eye plate: profile in the (b, z) plane, extruded along +a
eye = (cq.Workplane("YZ", origin=(a_eye_in, 0, 0))
       .moveTo(-EYE_W / 2, BAR_TOP)
       .lineTo(-EYE_W / 2, EYE_ZC)
       .threePointArc((0, EYE_ZC - EYE_R), (EYE_W / 2, EYE_ZC))
       .lineTo(EYE_W / 2, BAR_TOP)
       .close()
       .extrude(EYE_T))
eye = eye.cut(cyl_a(a_eye_in - 1, EYE_T + 2, 0, EYE_ZC, EYE_HOLE_D / 2))
eye = eye.cut(cyl_a(a_eye_in - 1, EYE_CB_DEPTH + 1, 0, EYE_ZC, EYE_CB_D / 2))

# flange housing: convex outline of top corners, ears and bottom tip
circles = [
    (FL_TOP_HW, FL_TOP, 0.0),
    (-FL_TOP_HW, FL_TOP, 0.0),
    (-EAR_C, FL_ZC, EAR_R),
    (0.0, TIP_ZC, TIP_R),
    (EAR_C, FL_ZC, EAR_R),
]
flange = hull_profile(cq.Workplane("YZ", origin=(a_fl_out, 0, 0)), circles).extrude(FL_T)
a_fl_in = a_fl_out + FL_T

# bearing seat recess on the inner face
flange = flange.cut(cyl_a(a_fl_in - RECESS_DEPTH, RECESS_DEPTH + 1, 0, FL_ZC,
                          RECESS_D / 2, seam_down=True))

# hexagonal nut pockets on the inner face at the ears
for sgn in (-1, 1):
    pocket = (cq.Workplane("YZ", origin=(a_fl_in - NUT_T, 0, 0)).center(sgn * EAR_C, FL_ZC)
              .polygon(6, NUT_AF / math.cos(math.radians(30))).extrude(NUT_T + 1))
    flange = flange.cut(pocket)

# bore and bolt holes
flange = flange.cut(cyl_a(a_fl_out - 1, FL_T + 2, 0, FL_ZC, BORE_D / 2, seam_down=True))
for sgn in (-1, 1):
    flange = flange.cut(cyl_a(a_fl_out - 1, FL_T + 2, sgn * EAR_C, FL_ZC, BOLT_D / 2,
                              seam_down=True))

fl_unit = fl_block.union(flange)                      # housing + end cap
eye_unit = eye_block.union(eye)
frame = bar.union(fl_unit).union(eye_unit)
frame = frame.rotate((0, 0, 0), (0, 0, 1), BAR_ANGLE)

# ---------------------------------------------------------------------------
# vertical rod at the bar centre
# ---------------------------------------------------------------------------
rod = (cq.Workplane("XY", origin=(0, 0, ROD_Z0)).circle(ROD_D / 2)
       .extrude(ROD_H - ROD_Z0)
       .rotate((0, 0, 0), (0, 0, 1), 90))      # keep the cylinder seam at the back
frame = frame.union(rod, clean=False)

# ---------------------------------------------------------------------------
# four standoff tiles
# ---------------------------------------------------------------------------
pads = []
pitch = TILE + TILE_GAP
for ix in (-0.5, 0.5):
    for iy in (-0.5, 0.5):
        cx = PAD_X + ix * pitch
        cy = PAD_Y + iy * pitch
        px, py = cx + PIN_OFF, cy - PIN_OFF
        tile = (cq.Workplane("XY").rect(TILE, TILE).extrude(TILE_T)
                .edges("|Z").fillet(TILE_R)
                .translate((cx, cy, 0)))
        pin = (cq.Workplane("XY", origin=(0, 0, TILE_T)).circle(PIN_D / 2)
               .extrude(PIN_TOP - TILE_T)
               .faces(">Z").edges().chamfer(PIN_CH)
               .rotate((0, 0, 0), (0, 0, 1), 90)        # seam to the back
               .translate((px, py, 0)))
        part = tile.union(pin)
        part = part.cut(cq.Workplane("XY", origin=(px, py, PIN_TOP - PIN_HOLE_DEPTH))
                        .circle(PIN_HOLE_D / 2).extrude(PIN_HOLE_DEPTH + 1))
        pads.append(part.val())

# final result: the bar assembly plus the four separate standoffs
solids = list(frame.val().Solids())
for p in pads:
    solids.extend(p.Solids())
result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])

VIEW = {"azimuth": 45, "elevation": 26}
